import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Split-keyboard style top frame (column staggered key well + thumb cluster)
# All layout values are expressed in key units (U) and scaled by the pitch.
# ---------------------------------------------------------------------------
U = 19.05             # key pitch [mm]
H = 0.563 * U         # frame height
R_TOP = 0.08 * U      # fillet on the outer top edge
CH_BOT = 0.04 * U     # small chamfer on the outer bottom edge
LIP = 0.10            # width of the outer lip around the bottom pocket (U)
POCKET_D = 0.185 * U  # depth of the bottom pocket (plate recess)
R_INNER = 0.5         # small round on the top edges of the key openings [mm]

# main key well: 6 columns x 4 rows, column stagger (in U)
N_COLS = 6
N_ROWS = 4
STAGGER = [0.0, 0.0, 0.255, 0.362, 0.255, 0.14]

# thumb cluster: two 1U cells (staggered) + one rotated 2U cell
THUMB_CELLS = [  # (x0, x1, y0, y1) in U
    (3.475, 4.49, -0.860, 0.162),
    (4.49, 5.505, -0.988, 0.048),
]
ROT_C = (6.325, -0.469)   # centre of the rotated 2U opening (U)
ROT_ANG = -30.0           # rotation of the 2U key (deg)
ROT_W, ROT_L = 1.0, 2.0   # opening size (U)
ROT_M_RIGHT = 0.425       # outer margins around the rotated opening (U)
ROT_M_TOP = 0.563
ROT_M_BOT = 0.48

# outer outline of the main well (U)
X_L = -0.395
Y_B = -0.40
X_R = 6.385
TOP_PTS = [(-0.395, 4.365), (1.320, 4.705), (2.857, 4.953), (3.924, 4.998),
           (4.929, 4.894), (5.461, 4.760), (5.997, 4.573), (6.385, 4.366)]
# thumb housing outline (U)
X_TH = 3.04               # left edge of the thumb housing
ARC_START_Y = -1.364      # where the concave lower arc meets the left edge
ARC_MID = (4.7, -1.581)   # a point on the concave lower arc

# vertical corner radii (U)
R_CORNER = 0.22
R_TH_CORNER = 0.24
R_ROT_RIGHT = 0.30
R_ROT_BOT = 0.25
R_CONCAVE_BIG = 0.57
R_CONCAVE_SMALL = 0.14

# blind screw holes in the pocket ceiling (U) and their size
HOLES = [(-0.12, -0.10), (3.12, -0.32), (3.318, -1.045), (6.963, 0.69),
         (4.578, 4.755), (3.321, 4.783), (-0.16, 4.137)]
HOLE_D = 0.08 * U
HOLE_DEPTH = 0.2 * U

_A = math.radians(ROT_ANG)
EX = (math.cos(_A), math.sin(_A))
EY = (-math.sin(_A), math.cos(_A))


def rot_pt(lx, ly):
    return (ROT_C[0] + EX[0] * lx + EY[0] * ly,
            ROT_C[1] + EX[1] * lx + EY[1] * ly)


def circle3(p1, p2, p3):
    ax, ay = p1
    bx, by = p2
    cx, cy = p3
    d = 2 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay)
          + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx)
          + (cx * cx + cy * cy) * (bx - ax)) / d
    return (ux, uy), math.hypot(ax - ux, ay - uy)


# the concave lower arc of the thumb housing (defined at zero inset)
ARC_C, ARC_R = circle3((X_TH, ARC_START_Y), ARC_MID,
                       rot_pt(ROT_W / 2 + ROT_M_RIGHT, -(ROT_L / 2 + ROT_M_BOT)))


def offset_polyline(pts, d):
    """offset a polyline of spline points to its right side (inwards)."""
    out = []
    n = len(pts)
    for i in range(n):
        p0 = pts[max(i - 1, 0)]
        p1 = pts[min(i + 1, n - 1)]
        tx, ty = p1[0] - p0[0], p1[1] - p0[1]
        ln = math.hypot(tx, ty)
        nx, ny = ty / ln, -tx / ln      # right-hand normal of a left->right curve
        out.append((pts[i][0] + nx * d, pts[i][1] + ny * d))
    return out


def outline_solid(inset, height):
    """outer outline of the frame shrunk by `inset` (U), extruded, corners rounded."""
    i = inset
    xl, yb, xr, xth = X_L + i, Y_B + i, X_R - i, X_TH + i
    # top spline, offset inwards, ends re-snapped to the side walls
    tp = offset_polyline(TOP_PTS, i)
    (x0, y0), (x1, y1) = tp[0], tp[1]
    tp[0] = (xl, y0 + (xl - x0) * (y1 - y0) / (x1 - x0))
    (x0, y0), (x1, y1) = tp[-1], tp[-2]
    tp[-1] = (xr, y0 + (xr - x0) * (y1 - y0) / (x1 - x0))
    # rotated thumb housing
    mr = ROT_W / 2 + ROT_M_RIGHT - i
    mt = ROT_L / 2 + ROT_M_TOP - i
    r_right = rot_pt(mr, mt)
    t = (xr - r_right[0]) / EX[0]
    concave = (xr, r_right[1] + EX[1] * t)
    # lower concave arc (radius grows when moving into the material)
    R = ARC_R + i
    cx, cy = ARC_C
    a_start = (xth, cy + math.sqrt(R * R - (xth - cx) ** 2))
    a_mid = (ARC_MID[0], cy + math.sqrt(R * R - (ARC_MID[0] - cx) ** 2))
    base = rot_pt(mr, 0.0)
    bx, by = base[0] - cx, base[1] - cy
    b = EY[0] * bx + EY[1] * by
    c = bx * bx + by * by - R * R
    ly = -b + math.sqrt(b * b - c)
    a_end = rot_pt(mr, ly)

    def P(p):
        return (p[0] * U, p[1] * U)

    wp = (cq.Workplane("XY")
          .moveTo(*P((xl, yb)))
          .lineTo(*P((xth, yb)))
          .lineTo(*P(a_start))
          .threePointArc(P(a_mid), P(a_end))
          .lineTo(*P(r_right))
          .lineTo(*P(concave))
          .lineTo(*P(tp[-1]))
          .spline([P(p) for p in reversed(tp[:-1])], includeCurrent=True)
          .close()
          .extrude(height))
    corners = [
        ((xl, yb), R_CORNER - i),
        ((xth, yb), R_CONCAVE_SMALL + i),
        (a_start, R_TH_CORNER - i),
        (a_end, R_ROT_BOT - i),
        (r_right, R_ROT_RIGHT - i),
        (concave, R_CONCAVE_BIG + i),
        (tp[-1], R_CORNER - i),
        (tp[0], R_CORNER - i),
    ]
    for (px, py), r in corners:
        sel = wp.edges("|Z").edges(cq.selectors.BoxSelector(
            (px * U - 0.1, py * U - 0.1, -1), (px * U + 0.1, py * U + 0.1, height + 1)))
        wp = sel.fillet(r * U)
    return wp


# main body with rounded outer top edge and a small bottom chamfer ------------
body = outline_solid(0.0, H)
body = body.faces(">Z").edges().fillet(R_TOP)
body = body.faces("<Z").edges().chamfer(CH_BOT)

# bottom pocket (plate recess) leaving a thin outer lip ------------------------
pocket = outline_solid(LIP, POCKET_D + 0.01).translate((0, 0, -0.01))

# key openings -------------------------------------------------------------------
cut = pocket
col_x = [0, 1, 2, 3, 4, 5, 6]
for k in range(N_COLS):
    xa, xb = col_x[k], col_x[k + 1]
    s = STAGGER[k]
    box = (cq.Workplane("XY")
           .center((xa + xb) / 2 * U, (s + N_ROWS / 2) * U)
           .rect((xb - xa) * U + (0.01 if k < N_COLS - 1 else 0), N_ROWS * U)
           .extrude(H + 2).translate((0, 0, -1)))
    cut = cut.union(box)

for (xa, xb, ya, yb) in THUMB_CELLS:
    box = (cq.Workplane("XY")
           .center((xa + xb) / 2 * U, (ya + yb) / 2 * U)
           .rect((xb - xa) * U, (yb - ya) * U)
           .extrude(H + 2).translate((0, 0, -1)))
    cut = cut.union(box)

rot_box = (cq.Workplane("XY")
           .rect(ROT_W * U, ROT_L * U)
           .extrude(H + 2).translate((0, 0, -1))
           .rotate((0, 0, 0), (0, 0, 1), ROT_ANG)
           .translate((ROT_C[0] * U, ROT_C[1] * U, 0)))
cut = cut.union(rot_box)

# blind holes going up from the pocket ceiling
holes = (cq.Workplane("XY").workplane(offset=POCKET_D - 0.01)
         .pushPoints([(x * U, y * U) for x, y in HOLES])
         .circle(HOLE_D / 2).extrude(HOLE_DEPTH))
cut = cut.union(holes)

frame = body.cut(cut)

# soften the top edges of the key openings (inner wires of the top face)
top_face = frame.faces(">Z").val()
inner_edges = [e for w in top_face.innerWires() for e in w.Edges()]
try:
    result = cq.Workplane("XY").add(frame.val().fillet(R_INNER, inner_edges))
except Exception:
    result = frame

VIEW = {"azimuth": 45, "elevation": 26}
